import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
R_SPHERE = 25.0          # radius of the spherical rim (barrel) = half of max diameter
THICK = 15.9             # overall thickness along Y (two parallel flat faces)
H = THICK / 2.0
R_FACE = math.sqrt(R_SPHERE ** 2 - H ** 2)   # radius of the flat faces

GROOVE_R0 = 10.5         # innermost ring groove radius
GROOVE_PITCH = 2.7       # radial pitch of the ring grooves
GROOVE_N = 5
GROOVE_RADII = [GROOVE_R0 + i * GROOVE_PITCH for i in range(GROOVE_N)]  # both faces
GROOVE_W = 0.3           # narrow, deep rectangular grooves
GROOVE_D = 0.7

SEAM_ANGLE = 130.0       # turn the revolved body so its seam sits out of sight

TEXT = "IJCK"            # engraved on the +Y face, upside down
TEXT_FONT = "DejaVu Serif"
TEXT_SIZE = 9.0
TEXT_DEPTH = 0.3
TEXT_ANGLE = 180.0       # in-plane rotation of the lettering
TEXT_XSCALE = 0.84       # horizontal condensing of the font
TEXT_CX, TEXT_CY = 0.0, -1.0  # centre of the lettering block (local x = +X, local y = -Z)

LOGO_DEPTH = 0.12        # small swoosh engraved on the top of the rim

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- revolve profile (r along X, axis along Y) ----------------
# narrow rectangular ring grooves are cut straight into the profile of both flat faces
def add_face(wp, y_face, sign, outward):
    """walk along a flat face, cutting a rectangular notch at every groove radius.
    sign = +1 for the +Y face (notch dips to -Y), -1 for the -Y face."""
    rs = GROOVE_RADII if outward else list(reversed(GROOVE_RADII))
    half = GROOVE_W / 2.0
    yd = y_face - sign * GROOVE_D
    for rg in rs:
        a, b = (rg - half, rg + half) if outward else (rg + half, rg - half)
        wp = wp.lineTo(a, y_face).lineTo(a, yd).lineTo(b, yd).lineTo(b, y_face)
    return wp

prof = cq.Workplane("XY").moveTo(0, -H)
prof = add_face(prof, -H, -1, True)
prof = prof.lineTo(R_FACE, -H)
prof = prof.threePointArc((R_SPHERE, 0), (R_FACE, H))
prof = add_face(prof, H, +1, False)
prof = prof.lineTo(0, H).close()

body = prof.revolve(360, (0, 0, 0), (0, 1, 0))
body = body.rotate((0, 0, 0), (0, 1, 0), SEAM_ANGLE)

# ---------------- engraved lettering on the +Y face ----------------
try:
    # lettering built flat on XY (extruded a little above the face so the cut is clean)
    letters = cq.Workplane("XY").text(TEXT, TEXT_SIZE, TEXT_DEPTH + 1.0, combine=False,
                                      font=TEXT_FONT, halign="center", valign="center").val()
    # condense the lettering horizontally (the engraved font is narrow)
    letters = letters.transformGeometry(
        cq.Matrix([[TEXT_XSCALE, 0, 0, 0], [0, 1, 0, 0], [0, 0, 1, 0], [0, 0, 0, 1]]))
    bb = letters.BoundingBox()
    letters = letters.translate(cq.Vector(-(bb.xmin + bb.xmax) / 2 + TEXT_CX,
                                          -(bb.ymin + bb.ymax) / 2 + TEXT_CY, -TEXT_DEPTH))
    # in-plane turn, then lay the XY lettering onto the +Y face
    # (local x -> +X, local y -> -Z, local z -> +Y : text reads upside down seen from +Y)
    letters = letters.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), TEXT_ANGLE - 180.0)
    letters = letters.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -90.0)
    letters = letters.translate(cq.Vector(0, H, 0))
    body = body.cut(cq.Workplane("XY").add(letters))
except Exception:
    pass

# ---------------- small swoosh logo engraved on the top of the rim ----------------
LOGO_DX = 0.2
logo_pts = [(x + LOGO_DX, y) for x, y in
            [(-12.7, -0.06), (-10.6, 0.05), (-8.1, -0.74), (-4.4, -0.95), (-0.2, 0.05),
             (-4.2, -1.17), (-7.5, -2.5), (-7.9, -1.7), (-10.7, -1.1)]]
logo_prism = (cq.Workplane("XY").workplane(offset=R_SPHERE - 6)
              .polyline(logo_pts).close().extrude(8))
shell = (cq.Workplane("XY").sphere(R_SPHERE + 1)
         .cut(cq.Workplane("XY").sphere(R_SPHERE - LOGO_DEPTH)))
body = body.cut(logo_prism.intersect(shell))

result = body
